import cadquery as cq
import math

# ---------------- driving dimensions (mm) ----------------
FL_R = 7.0            # flange outer radius
RIM_T = 0.75          # cylindrical rim thickness of the flange
DOME_H = 1.0          # height of the domed cap above the rim
DOME_FLAT_R = 3.2     # radius where the dome starts to fall off
TUBE_L = 13.38        # tube length (flange underside to tip)
WALL = 0.75           # tube wall thickness at the tip
R_IN_ROOT = 4.27      # bore radius at the bore floor (bore is a drafted cone)
# outer profile of the (slightly flared) tube: (radius, distance from flange)
TUBE_PROFILE = [(4.91, 0.0), (4.94, 3.0), (5.11, 5.2), (5.26, 8.0), (5.32, 10.5), (5.29, TUBE_L)]
HOLE_D = 2.48         # centre through hole
CSK_D = 4.1           # countersink diameter on the dome face
CSK_ANGLE = 60.0      # countersink included angle (deg)
BORE_FLOOR = -0.35    # axial position of the bore floor (0 = flange underside)
SLOT_L = 8.8          # V-slot length from tip
SLOT_W_TIP = 2.47     # V-slot width at tip
SLOT_W_ROOT = 1.14    # V-slot width at closed end
N_SLOTS = 4
SEAM_ANGLE = 230.0    # angular position of the revolve seam (cosmetic only)

# Axis of the part = Y. Flange at +Y (y = 0 .. RIM_T + DOME_H), tube toward -Y.
# Half profile drawn in the XY plane (x = radius, y = axial) and revolved about Y.
y_rim = RIM_T
y_top = RIM_T + DOME_H
r_h = HOLE_D / 2.0
r_cs = CSK_D / 2.0
y_cs = y_top - (r_cs - r_h) / math.tan(math.radians(CSK_ANGLE / 2.0))

# dome: flat centre falling off along a circular-arc law toward the rim edge;
# drawn as one smooth spline so the whole cap is a single face
d = FL_R - DOME_FLAT_R
arc_R = (d * d + DOME_H * DOME_H) / (2.0 * DOME_H)


def dome_y(r):
    t = max(0.0, r - DOME_FLAT_R)
    return y_top - (arc_R - math.sqrt(arc_R ** 2 - t * t))


dome_pts = [(r, dome_y(r)) for r in (4.0, 5.0, 6.0)] + [(FL_R, y_rim)]
dome_end_slope = d / math.sqrt(arc_R ** 2 - d * d)

outer = [(r, -z) for r, z in TUBE_PROFILE]
r_in_tip = TUBE_PROFILE[-1][0] - WALL
tan_root = (0.0, -1.0)
tan_tip = (-0.03, -1.0)

prof = (
    cq.Workplane("XY")
    .moveTo(r_cs, y_top)
    .spline(dome_pts, tangents=[(1.0, 0.0), (1.0, -dome_end_slope)], includeCurrent=True)
    .lineTo(FL_R, 0)
    .lineTo(outer[0][0], 0)
    .spline(outer[1:], tangents=[tan_root, tan_tip], includeCurrent=True)
    .lineTo(r_in_tip, -TUBE_L)
    .lineTo(R_IN_ROOT, BORE_FLOOR)
    .lineTo(r_h, BORE_FLOOR)
    .lineTo(r_h, y_cs)
    .close()
)
body = prof.revolve(360, (0, 0, 0), (0, 1, 0))
# revolve seam starts at +X; turn it to a side no standard view looks at
body = body.rotate((0, 0, 0), (0, 1, 0), 360.0 - SEAM_ANGLE)

# V-shaped slots, open at the tip, at 0/90/180/270 deg around the axis
ext = 1.0
half_tip = SLOT_W_TIP / 2 + (SLOT_W_TIP - SLOT_W_ROOT) / 2 / SLOT_L * ext
for i in range(N_SLOTS):
    ang = i * 360.0 / N_SLOTS
    pts = [
        (-TUBE_L - ext, -half_tip),
        (-TUBE_L + SLOT_L, -SLOT_W_ROOT / 2),
        (-TUBE_L + SLOT_L, SLOT_W_ROOT / 2),
        (-TUBE_L - ext, half_tip),
    ]
    wp = cq.Workplane(cq.Plane(origin=(0, 0, 0), xDir=(0, 1, 0), normal=(1, 0, 0)))
    cutter = wp.polyline(pts).close().extrude(FL_R)
    cutter = cutter.rotate((0, 0, 0), (0, 1, 0), ang)
    body = body.cut(cutter)

result = body
